import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 20.0            # rod diameter
L = 200.0           # overall length
NECK_D = 10.0       # minimum diameter at the neck groove
FLANK_ANG = 32.0    # groove flank angle, measured from the rod axis (deg)
ROOT_R = 8.0        # concave blend radius at the groove root
SHOULDER_R = 10.0   # convex blend radius at the groove shoulders
NECK_X = 0.0        # axial position of the neck (rod centre = 0)
SEAM_ANG = -50.0    # roll of the revolve seam about the axis (cosmetic only)

# ---------------- derived groove geometry ----------------
R = D / 2.0
r = NECK_D / 2.0
d = R - r
th = math.radians(FLANK_ANG)
s, c = math.sin(th), math.cos(th)

# tangent point root-arc / flank (right half, x measured from the neck)
tr = (ROOT_R * s, r + ROOT_R * (1.0 - c))
# where the shoulder blend meets the cylinder (= groove half width)
xs = (d - (ROOT_R + SHOULDER_R) * (1.0 - c)) / math.tan(th) + (ROOT_R + SHOULDER_R) * s
# tangent point flank / shoulder-arc
ts = (xs - SHOULDER_R * s, R - SHOULDER_R * (1.0 - c))
# mid points of the shoulder arcs (for three-point arcs)
am = math.pi / 2 + th / 2
sh_r = (xs + SHOULDER_R * math.cos(am), R - SHOULDER_R + SHOULDER_R * math.sin(am))
sh_l = (-sh_r[0], sh_r[1])

x0, x1 = -L / 2.0 - NECK_X, L / 2.0 - NECK_X   # rod ends relative to the neck

# half cross-section in the XY plane (y = radius), revolved about the X axis
prof = (cq.Workplane("XY", origin=(NECK_X, 0, 0))
        .moveTo(x0, 0)
        .lineTo(x0, R)
        .lineTo(-xs, R)
        .threePointArc(sh_l, (-ts[0], ts[1]))
        .lineTo(-tr[0], tr[1])
        .threePointArc((0.0, r), (tr[0], tr[1]))
        .lineTo(ts[0], ts[1])
        .threePointArc(sh_r, (xs, R))
        .lineTo(x1, R)
        .lineTo(x1, 0)
        .close())

rod = prof.revolve(360.0, (0, 0, 0), (1, 0, 0))
# the part is axisymmetric: rolling it only moves the revolve seam out of sight
result = rod.rotate((0, 0, 0), (1, 0, 0), SEAM_ANG)
VIEW = {"azimuth": 45, "elevation": 26}
